import cadquery as cq

# ---------------------------------------------------------------------------
# 3 x 3 set of loose square tiles (rounded corners) laid out on a regular grid
# with a narrow gap between them; every tile carries one shallow round pocket
# (e.g. for a magnet) in the middle of its underside.
# ---------------------------------------------------------------------------

# ---- driving dimensions (mm) ----
N_X = 3            # tiles along X
N_Y = 3            # tiles along Y
TILE_W = 50.0      # tile edge length (square tiles)
GAP = 2.0          # clear gap between neighbouring tiles
CORNER_R = 9.5     # plan-view corner radius of each tile
THICK = 3.5        # tile thickness
POCKET_D = 10.0    # round pocket in the underside of each tile
POCKET_DEPTH = 2.0 # pocket depth (from the underside)

PITCH = TILE_W + GAP

# tile centres of the rectangular pattern, centred on the origin
centres = [
    ((i - (N_X - 1) / 2.0) * PITCH, (j - (N_Y - 1) / 2.0) * PITCH)
    for i in range(N_X)
    for j in range(N_Y)
]

# one tile: rounded-square plate with the underside pocket
tile = (
    cq.Workplane("XY")
    .sketch()
    .rect(TILE_W, TILE_W)
    .vertices()
    .fillet(CORNER_R)
    .finalize()
    .extrude(THICK)
    .faces("<Z")
    .workplane(centerOption="CenterOfBoundBox")
    .hole(POCKET_D, POCKET_DEPTH)
)
tile_solid = tile.val()

# rectangular pattern of separate tiles (they do not touch: GAP > 0)
solids = [tile_solid.translate(cq.Vector(x, y, 0.0)) for (x, y) in centres]
result = cq.Workplane("XY").newObject([cq.Compound.makeCompound(solids)])

VIEW = {"azimuth": 45, "elevation": 26}
